import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_SPAN_Y = 300.0          # overall extent of the plate along Y
THICKNESS = 5.7               # plate thickness
HOLE_D = 6.6                  # diameter of the 8 plain through holes
KINK_ROUND = 3.0              # blend length (drawing units) at soft kinks

# Outline digitised from the plan view (drawing units, x right, y down).
#   ("L", pt)            straight edge to pt
#   ("K", [pts], r)      one smooth edge following the polyline through pts,
#                        its interior kinks blended over length r
#   ("S", [pts])         interpolating spline through pts
#   ("A", mid, end)      three-point arc
START = (45.9, 279.2)                                   # top-left corner
OUTLINE = [
    ("K", [(77.7, 275.6), (107.0, 275.9)], KINK_ROUND),  # top-left edge
    ("L", (109.6, 271.5)),                              # raised tab
    ("L", (138.4, 271.25)),
    ("L", (144.0, 275.2)),
    ("L", (178.5, 277.5)),
    ("L", (182.8, 297.0)),                              # step down
    ("K", [(202.2, 294.4), (241.5, 298.0)], KINK_ROUND),  # top-right edge
    ("K", [(244.6, 327.3), (243.6, 372.0), (243.1, 414.0),
           (240.8, 447.8)], 6.0),                       # right edge
    ("K", [(207.3, 451.5), (180.2, 451.4)], KINK_ROUND),  # bottom-right edge
    ("L", (175.6, 462.9)),                              # notch
    ("L", (148.7, 461.7)),
    ("L", (130.7, 479.1)),                              # chamfer
    ("K", [(103.6, 483.4), (54.2, 507.9)], KINK_ROUND),   # bottom-left edge
    ("K", [(33.4, 484.0), (31.0, 473.5), (15.4, 448.5)], 4.5),  # relief
    # (15.4, 448.5) is the left-most point; from there one smooth edge runs
    # back up to the top-left corner (per-point blend lengths in 3rd slot)
    ("K", [(32.6, 429.9, 3.0), (35.8, 414.7, 3.0), (30.2, 397.2, 4.0),
           (28.7, 380.0, 8.0), (30.3, 345.0, 10.0), (34.8, 308.3, 6.0),
           START], 4.0),                                # curved left edge
]
HOLES = [
    (113.0, 283.3), (190.4, 307.6), (231.7, 351.7), (220.6, 438.8),
    (132.5, 461.2), (44.0, 474.5), (44.6, 404.8), (45.9, 316.0),
]

# bounding box of the digitised outline -> centre & scale
_all = [START]
for seg in OUTLINE:
    if seg[0] == "L":
        _all.append(seg[1])
    elif seg[0] in ("K", "S"):
        _all.extend(seg[1])
    else:
        _all.extend([seg[1], seg[2]])
_xs = [p[0] for p in _all]
_ys = [p[1] for p in _all]
CX = (min(_xs) + max(_xs)) / 2.0
CY = (min(_ys) + max(_ys)) / 2.0
SCALE = PLATE_SPAN_Y / (max(_ys) - min(_ys))


def mm(p):
    """drawing units -> model mm (Y flipped so +Y is up the plan view)"""
    return ((p[0] - CX) * SCALE, -(p[1] - CY) * SCALE)


def V(p):
    q = mm(p[:2])
    return cq.Vector(q[0], q[1], 0.0)


def _unit(a, b):
    dx, dy = b[0] - a[0], b[1] - a[1]
    L = math.hypot(dx, dy)
    return (dx / L, dy / L), L


def blended_polyline_edge(pts, r):
    """Single smooth spline edge that runs straight along the legs of the
    polyline pts and rounds each interior kink over a length ~r (or over
    the per-point length given as a third tuple element); Hermite
    interpolation with prescribed tangents."""
    P = [pts[0][:2]]
    T = [_unit(pts[0], pts[1])[0]]
    for i in range(1, len(pts) - 1):
        A, K, B = pts[i - 1][:2], pts[i][:2], pts[i + 1][:2]
        rk = pts[i][2] if len(pts[i]) > 2 else r
        d1, L1 = _unit(A, K)
        d2, L2 = _unit(K, B)
        r1, r2 = min(rk, 0.45 * L1), min(rk, 0.45 * L2)
        p1 = (K[0] - r1 * d1[0], K[1] - r1 * d1[1])
        p2 = (K[0] + r2 * d2[0], K[1] + r2 * d2[1])
        m = (0.25 * p1[0] + 0.5 * K[0] + 0.25 * p2[0],
             0.25 * p1[1] + 0.5 * K[1] + 0.25 * p2[1])
        tm, _ = _unit(p1, p2)
        P += [p1, m, p2]
        T += [d1, tm, d2]
    P.append(pts[-1][:2])
    T.append(_unit(pts[-2], pts[-1])[0])
    # arc-length-like parametrisation (unit tangents, chord-length
    # parameters) keeps the curve speed uniform along the straight legs
    vs = [V(p) for p in P]
    params = [0.0]
    for a, b in zip(vs[:-1], vs[1:]):
        params.append(params[-1] + (b - a).Length)
    # drawing y points down -> flip tangent y
    return cq.Edge.makeSpline(
        vs,
        tangents=[cq.Vector(t[0], -t[1], 0) for t in T],
        parameters=params,
        scale=False,
    )


# ---------------- plate outline ----------------
edges = []
prev = START
for seg in OUTLINE:
    kind = seg[0]
    if kind == "L":
        edges.append(cq.Edge.makeLine(V(prev), V(seg[1])))
        prev = seg[1]
    elif kind == "K":
        edges.append(blended_polyline_edge([prev] + list(seg[1]), seg[2]))
        prev = seg[1][-1]
    elif kind == "S":
        edges.append(cq.Edge.makeSpline([V(prev)] + [V(p) for p in seg[1]]))
        prev = seg[1][-1]
    else:
        edges.append(cq.Edge.makeThreePointArc(V(prev), V(seg[1]), V(seg[2])))
        prev = seg[2]
if (abs(prev[0] - START[0]) + abs(prev[1] - START[1])) > 1e-9:
    edges.append(cq.Edge.makeLine(V(prev), V(START)))  # close the loop

outline_wire = cq.Wire.assembleEdges(edges)
plate_face = cq.Face.makeFromWires(outline_wire)
plate_solid = cq.Solid.extrudeLinear(plate_face, cq.Vector(0, 0, THICKNESS))

# ---------------- through holes ----------------
plate = (
    cq.Workplane("XY").add(plate_solid)
    .faces(">Z").workplane(centerOption="ProjectedOrigin")
    .pushPoints([mm(h) for h in HOLES])
    .hole(HOLE_D)
)

result = plate
VIEW = {"azimuth": 45, "elevation": 26}
